import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
BASE_W = 80.0          # base width along X (square mounting area)
BASE_SQ = 80.0         # depth of square mounting area along Y
BASE_T = 7.6           # base plate thickness

UP_W = 43.6            # upright plate width (X)
UP_T = 7.6             # upright plate thickness (Y), sits behind the square area
UP_H = 23.0            # upright height above base top

HOLE_D = 6.5           # corner mounting holes
HOLE_INSET = 11.0      # hole centre distance from square edges

CONE_D1 = 31.5         # raised frustum base diameter
CONE_D2 = 14.4         # raised frustum top diameter
CONE_H = 5.1           # raised frustum height
CONE_BASE_FILLET = 1.5 # concave blend frustum -> base top
CONE_TOP_FILLET = 1.0  # convex round frustum flank -> top land
HOLE_EDGE_FILLET = 0.6 # round on the top edge of the centre hole
CENTER_HOLE_D = 12.4   # through hole in frustum
CONE_SEAM_ANGLE = 135.0  # orientation of the frustum parametric seam (cosmetic)

RECESS_D = 44.0        # circular recess on the underside
RECESS_DEPTH = 3.3

CB_D = 19.0            # counterbore on upright front face
CB_DEPTH = 4.0
TD_D = 10.5            # teardrop through hole in upright
TD_Z = UP_H / 2.0      # hole centre height above base top
TD_TIP = 1.33          # teardrop tip distance from hole centre, in radii

# ---------------- derived ----------------
y_front = -BASE_SQ / 2.0
base_len = BASE_SQ + UP_T

# base plate
base = (
    cq.Workplane("XY")
    .box(BASE_W, base_len, BASE_T, centered=(True, False, False))
    .translate((0, y_front, 0))
)

# upright plate at the back edge, flush with back face
upright = (
    cq.Workplane("XY")
    .box(UP_W, UP_T, UP_H, centered=(True, False, False))
    .translate((0, BASE_SQ / 2.0, BASE_T))
)

# raised frustum in the centre of the square area
cone = cq.Workplane("XY").add(
    cq.Solid.makeCone(
        CONE_D1 / 2.0, CONE_D2 / 2.0, CONE_H,
        cq.Vector(0, 0, BASE_T), cq.Vector(0, 0, 1)
    ).rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), CONE_SEAM_ANGLE)
)

part = base.union(upright).union(cone)


def _circ_edges(shape, z, rad):
    """circular edges centred on the Z axis at height z with radius rad"""
    out = []
    for e in shape.Edges():
        if e.geomType() != "CIRCLE":
            continue
        c = e.Center()
        if abs(c.z - z) > 1e-4 or abs(c.x) > 1e-4 or abs(c.y) > 1e-4:
            continue
        if abs(e.radius() - rad) > 1e-3:
            continue
        out.append(e)
    return out


# blend the frustum foot and round its top rim
s0 = part.val()
s0 = s0.fillet(CONE_BASE_FILLET, _circ_edges(s0, BASE_T, CONE_D1 / 2.0))
s0 = s0.fillet(CONE_TOP_FILLET, _circ_edges(s0, BASE_T + CONE_H, CONE_D2 / 2.0))
part = cq.Workplane("XY").add(s0)

# centre through hole
part = part.cut(
    cq.Workplane("XY").circle(CENTER_HOLE_D / 2.0).extrude(BASE_T + CONE_H + 2).translate((0, 0, -1))
)

# round the top edge of the centre hole
s1 = part.val()
s1 = s1.fillet(HOLE_EDGE_FILLET, _circ_edges(s1, BASE_T + CONE_H, CENTER_HOLE_D / 2.0))
part = cq.Workplane("XY").add(s1)

# underside circular recess
part = part.cut(
    cq.Workplane("XY").circle(RECESS_D / 2.0).extrude(RECESS_DEPTH + 0.001).translate((0, 0, -0.001))
)

# four corner holes
off = BASE_SQ / 2.0 - HOLE_INSET
pts = [(sx * (BASE_W / 2.0 - HOLE_INSET), sy * off) for sx in (-1, 1) for sy in (-1, 1)]
part = part.cut(
    cq.Workplane("XY").pushPoints(pts).circle(HOLE_D / 2.0).extrude(BASE_T + 2).translate((0, 0, -1))
)

# counterbore on the upright front face (-Y side)
zc = BASE_T + TD_Z
cb = (
    cq.Workplane("XZ", origin=(0, BASE_SQ / 2.0, 0))
    .center(0, zc)
    .circle(CB_D / 2.0)
    .extrude(-CB_DEPTH)
)
part = part.cut(cb)

# teardrop through hole (tip pointing up)
r = TD_D / 2.0
tip = TD_TIP * r
th = math.acos(r / tip)            # tangent point angle from vertical
tx, tz = r * math.sin(th), r * math.cos(th)
td = (
    cq.Workplane("XZ", origin=(0, BASE_SQ / 2.0 - 1.0, 0))
    .center(0, zc)
    .moveTo(-tx, tz)
    .lineTo(0, tip)
    .lineTo(tx, tz)
    .threePointArc((0, -r), (-tx, tz))
    .close()
    .extrude(-(UP_T + 2.0))
)
part = part.cut(td)

result = part

VIEW = {"azimuth": 45, "elevation": 26}
